import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT = 50.0          # outer radius of the hemispherical dome
WALL = 3.7            # dome wall thickness
BOSS_D = 20.5         # outer diameter of the central boss
THREAD_D = 13.0       # tapped hole in the boss (thread modelled as plain bore)
THREAD_DEPTH = 30.0   # depth of the tapped hole from the open face
TOP_HOLE_D = 3.3      # small blind hole at the crown
TOP_HOLE_DEPTH = 10.0 # depth of the crown hole (it does not reach the tapped hole)
RIB_T = 3.0           # rib thickness
RIB_COUNT = 3
RIB_ANGLE0 = 90.0     # angle of the first rib (deg, from +X in the XY plane)
OUTER_SEAM_ANGLE = 135.0   # where the sphere's parametric seam sits (cosmetic only)

R_IN = R_OUT - WALL
ORIGIN, Z_AXIS = (0, 0, 0), (0, 0, 1)


def sphere(radius, lat_from, lat_to, seam_angle):
    """Spherical solid (latitude band lat_from..lat_to) centred on the origin,
    axis along Z, with its parametric seam turned to seam_angle."""
    s = cq.Solid.makeSphere(radius, angleDegrees1=lat_from, angleDegrees2=lat_to)
    return cq.Workplane("XY").add(s).rotate(ORIGIN, Z_AXIS, seam_angle)


# ---------------- dome shell ----------------
outer_hemi = sphere(R_OUT, 0, 90, OUTER_SEAM_ANGLE)
cavity = sphere(R_IN, -90, 90, RIB_ANGLE0)        # inner seam hides inside a rib
shell = outer_hemi.cut(cavity)

# ---------------- central boss ----------------
boss = cq.Workplane("XY").circle(BOSS_D / 2.0).extrude(R_OUT)

# ---------------- radial ribs (full height, flush with the open face) ----------------
ribs = None
for i in range(RIB_COUNT):
    ang = RIB_ANGLE0 + i * 360.0 / RIB_COUNT
    rib = (
        cq.Workplane("XY")
        .center(R_OUT / 2.0, 0)
        .rect(R_OUT, RIB_T)
        .extrude(R_OUT)
        .rotate(ORIGIN, Z_AXIS, ang)
    )
    ribs = rib if ribs is None else ribs.union(rib)

# trim boss and ribs so that they end inside the dome wall
trim = sphere(R_IN + 0.5 * WALL, 0, 90, RIB_ANGLE0)
inner_struct = boss.union(ribs).intersect(trim)

body = shell.union(inner_struct)

# ---------------- holes ----------------
tapped = cq.Workplane("XY").circle(THREAD_D / 2.0).extrude(THREAD_DEPTH)
top_hole = (
    cq.Workplane("XY")
    .workplane(offset=R_OUT - TOP_HOLE_DEPTH)
    .circle(TOP_HOLE_D / 2.0)
    .extrude(TOP_HOLE_DEPTH + 5.0)
)

result = body.cut(tapped).cut(top_hole).clean()

VIEW = {"azimuth": 45, "elevation": 26}
